"""Bent thick liftarm, 7 holes (4 - 4, shared corner hole), 60 deg bend.

The beam lies in the XZ plane, holes run along Y.  Both faces carry the
typical liftarm pattern: an outer rim, recessed hole tubes tied together by
centre-line ribs and small connectors to the rim, and deep pockets down to a
thin central web.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
P = 8.0            # hole pitch
W = 8.0            # in-plane beam width
T = 8.0            # thickness along hole axis (Y)
N_ARM = 3          # pitches per arm (4 holes per arm, corner hole shared)
A_LOW = 15.0       # direction of lower arm (deg, from left end toward corner)
A_UP = 75.0        # direction of upper arm (deg, from corner toward top end)
RIM = 0.7          # outer rim wall thickness
REC = 0.65         # recess of tube / rib faces below the rim face
POCKET_D = 3.6     # pocket depth measured from the rim face (web = T - 2*D)
HOLE_D = 4.0       # pin hole diameter
TUBE_D = 5.5       # outer diameter of hole tubes
RIB_W = 0.85       # width of centre-line ribs and rim connectors
CORNER_CH = 0.6    # width of the flat on the inner rim corner
WEB_W1 = 0.6       # corner web width at the rim
WEB_W2 = 0.87      # corner web width at the tube
EDGE_R = 0.15      # small round on the outer perimeter edges of both faces

R = W / 2.0
RP = R - RIM       # pocket half width
RT = TUBE_D / 2.0
YI = -T / 2 + REC  # recessed face level of tubes / ribs (front side)
HI = T - 2 * REC   # height of tubes / ribs


def pol(r, ang):
    a = math.radians(ang)
    return (r * math.cos(a), r * math.sin(a))


def add2(p, q):
    return (p[0] + q[0], p[1] + q[1])


# hole centres in the XZ plane (x, z)
low = [pol(-k * P, A_LOW) for k in range(N_ARM + 1)]   # low[0] = corner
up = [pol(k * P, A_UP) for k in range(N_ARM + 1)]      # up[0] = corner
centres = low[::-1] + up[1:]

# inner corner of the bend
BIS = (A_LOW + 180.0 + A_UP) / 2.0            # inner bisector direction
HALF_BEND = math.radians((A_UP - A_LOW) / 2.0)
Q_IN = RP / math.cos(HALF_BEND)               # pocket inner corner distance
T_CH = CORNER_CH / 2.0 * math.tan(HALF_BEND)  # depth of the corner flat


def xz(y0, h):
    """XZ workplane whose extrusion of height h spans y0 .. y0 + h"""
    return cq.Workplane("XZ", origin=(0, y0 + h, 0))


def slot_solid(p1, p2, r, y0, h):
    """stadium around segment p1-p2 (XZ), radius r, spanning y0..y0+h in Y"""
    dx, dz = p2[0] - p1[0], p2[1] - p1[1]
    L = math.hypot(dx, dz)
    ang = math.degrees(math.atan2(dz, dx))
    cx, cz = (p1[0] + p2[0]) / 2.0, (p1[1] + p2[1]) / 2.0
    return xz(y0, h).center(cx, cz).slot2D(L + 2 * r, 2 * r, ang).extrude(h)


def bar(p1, p2, w, y0, h):
    """rectangular rib from p1 to p2 (XZ), width w, spanning y0..y0+h"""
    dx, dz = p2[0] - p1[0], p2[1] - p1[1]
    L = math.hypot(dx, dz)
    ang = math.degrees(math.atan2(dz, dx))
    cx, cz = (p1[0] + p2[0]) / 2.0, (p1[1] + p2[1]) / 2.0
    return (xz(y0, h).transformed(offset=(cx, cz, 0), rotate=(0, 0, ang))
            .rect(L, w).extrude(h))


def cyl(c, r, y0, h):
    return xz(y0, h).center(c[0], c[1]).circle(r).extrude(h)


def poly(pts, y0, h):
    return xz(y0, h).polyline(pts).close().extrude(h)


def profile(r, y0, h):
    """beam outline (two stadiums) offset to 'radius' r"""
    return slot_solid(low[-1], low[0], r, y0, h).union(
        slot_solid(up[0], up[-1], r, y0, h))


def on_bis(d, lat):
    """point at distance d along the inner bisector, offset lat sideways"""
    return add2(pol(d, BIS), pol(lat, BIS + 90.0))


# ---------------- outer body ----------------
body = profile(R, -T / 2, T)
if EDGE_R > 0:
    body = body.faces("<Y or >Y").edges().fillet(EDGE_R)

# ---------------- pockets on both faces ----------------
for y0 in (-T / 2 - 0.01, T / 2 - POCKET_D):
    body = body.cut(profile(RP, y0, POCKET_D + 0.01))
    # small flat on the convex inner corner of the rim
    tri = [pol(Q_IN - 0.15, BIS),
           on_bis(Q_IN + T_CH, CORNER_CH / 2.0),
           on_bis(Q_IN + T_CH, -CORNER_CH / 2.0)]
    body = body.cut(poly(tri, y0, POCKET_D + 0.01))


# ---------------- tubes, ribs and connectors (recessed below rim face) ----
def connector(c, ang, kinds=("line", "line")):
    """bar of width RIB_W tying a tube (centre c) to the rim in direction ang,
    with rounded (U-shaped) ends of the narrow tube/rim gap on both sides.
    kinds[i] describes the rim on side +v / -v: 'line' (straight side wall)
    or 'arc' (rim concentric with the tube, i.e. at a rounded end)."""
    w2 = RIB_W / 2.0
    u = pol(1.0, ang)
    v = pol(1.0, ang + 90.0)
    sides = []
    for sgn, kind in zip((1.0, -1.0), kinds):
        r = 0.3
        for _ in range(30):
            L = w2 + r
            a = math.sqrt(RT * RT - L * L)
            b = RP if kind == "line" else math.sqrt(RP * RP - L * L)
            r = (b - a) / 2.0
        sides.append((sgn, w2 + r, (a + b) / 2.0, r, a, b))
    r0 = min(sd[4] for sd in sides) - 0.4
    r1 = max(sd[5] for sd in sides) + 0.3

    def p2(rad, lat):
        return (c[0] + u[0] * rad + v[0] * lat, c[1] + u[1] * rad + v[1] * lat)

    lp, lm = sides[0][1], sides[1][1]
    shape = poly([p2(r0, -lm), p2(r1, -lm), p2(r1, lp), p2(r0, lp)], YI, HI)
    for sgn, L, m, r, a, b in sides:
        shape = shape.cut(cyl(p2(m, sgn * L), r + 0.015, YI - 0.1, HI + 0.2))
    return shape


parts = [cyl(c, RT, YI, HI) for c in centres]

for arm, ang in ((low, A_LOW + 180.0), (up, A_UP)):
    # centre-line rib running through all tubes of the arm
    parts.append(bar(arm[0], arm[-1], RIB_W, YI, HI))
    # connector at the rounded end (apex)
    parts.append(connector(arm[-1], ang, ("arc", "arc")))
    # connectors from each intermediate tube to both side walls
    for c in arm[1:-1]:
        for s in (90.0, -90.0):
            parts.append(connector(c, ang + s))
    # end tube side connectors sit where the end arc meets the side wall
    parts.append(connector(arm[-1], ang + 90.0, ("line", "arc")))
    parts.append(connector(arm[-1], ang - 90.0, ("arc", "line")))


# corner tube: tapered web to the flat on the inner rim corner ...
def hw_web(d):
    f = (Q_IN + T_CH - d) / (Q_IN + T_CH - RT)
    return WEB_W1 / 2 + (WEB_W2 - WEB_W1) / 2 * f


d_out, d_in = Q_IN + T_CH + 0.1, RT - 0.5
parts.append(poly([on_bis(d_out, hw_web(d_out)), on_bis(d_out, -hw_web(d_out)),
                   on_bis(d_in, -hw_web(d_in)), on_bis(d_in, hw_web(d_in))],
                  YI, HI))
# ... and a connector to the rounded outer corner
parts.append(connector((0.0, 0.0), BIS + 180.0, ("arc", "arc")))

inner = parts[0]
for p in parts[1:]:
    inner = inner.union(p)
body = body.union(inner)

# ---------------- pin holes ----------------
for c in centres:
    body = body.cut(cyl(c, HOLE_D / 2, -T / 2 - 1, T + 2))

result = body
